import math
import cadquery as cq

# =====================================================================
# Snap-on cover disc: front recess with a flush central boss (4 holes),
# 8 latch tabs and 4 detent nubs on the rim wall, one slot across the
# rim, and a domed / rolled back with a central hub pocket.
# Disc axis = Y, open front face at Y = 0 (facing -Y), back towards +Y.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
R = 50.0            # outer radius of the disc
T = 18.3            # overall thickness (along +Y)
RI = 44.6           # inner radius of the rim (recess wall)
D_REC = 11.5        # depth of the front recess (floor plane Y)
RB = 19.0           # radius of the central front boss
BOSS_FRONT = 0.0    # Y of the boss front face (flush with rim)
HOLE_OFF = 5.5      # hole centre offset in X and Z
HOLE_R = 2.65       # hole radius
HOLE_FIL = 0.5      # round on the hole mouths

CYL_LEN = 12.3      # axial length of the straight outer cylinder
R_CREST = 34.5      # radius where the back roll reaches full thickness
HUB_Y = 8.0         # Y of the flat back hub face (floor of the hub pocket)
DISH_R = 12.3       # radius of the hub pocket wall (where the back dome ends)
DISH_Y = 10.8       # Y where the back dome meets the hub pocket wall
DISH_FIL = 1.2      # fillet dome -> pocket wall
HUB_FIL = 1.2       # fillet pocket wall -> hub face

# rim slot (notch) across the rim, centred on 112.5 deg
SLOT_ANG = 112.5
SLOT_W = 32.0
SLOT_D = 5.2
SLOT_FIL = 2.0      # round between slot floor and slot end walls
SLOT_R0 = RI - 6.0  # inner start radius of the slot cutter (inside the recess)

# latch tabs on the rim inner wall
N_TABS = 8
TAB_BASE_W = 8.4    # width of the tab where it meets the rim wall
TAB_TIP_R = 3.0     # radius of the rounded tab tip (tangent to the flanks)
TAB_P = 5.4         # radial protrusion
TAB_FRONT = 7.0     # Y of tab front face

# small half-round detent nubs at the front edge of the rim wall
RIB_R = 1.6
RIB_L = 2.0         # axial length of the nubs
RIB_ANGS = [67.5, 157.5, 247.5, 337.5]

# edge treatment
ROLL_FIL = 1.5      # outer cylinder -> back roll
RIM_OUT_FIL = 0.6   # rim outer front edge
RIM_IN_FIL = 0.6    # rim inner front edge (and nubs)
FLOOR_FIL = 1.5     # recess floor -> rim wall and tabs
BOSS_BASE_FIL = 2.0
BOSS_FRONT_FIL = 1.0

VIEW = {"azimuth": 45, "elevation": 26}


def sel_circ(wp, radius, y, tol=0.15):
    """circular edges (centred on the Y axis) of given radius at axial position y"""
    out = []
    for e in wp.edges().vals():
        if e.geomType() != "CIRCLE":
            continue
        p = e.positionAt(0.0)
        c = e.Center()
        r = math.hypot(p.x - c.x, p.z - c.z)
        if abs(r - radius) < tol and abs(p.y - y) < tol and abs(c.x) < 1e-3 and abs(c.z) < 1e-3:
            out.append(e)
    return out


def fillet_circ(wp, radius, y, f):
    edges = sel_circ(wp, radius, y)
    if not edges:
        return wp
    return wp.newObject(edges).fillet(f)


def planar_edges(wp, y, rmin, rmax):
    """all edges lying in the plane Y=y whose midpoint radius is within [rmin, rmax]"""
    out = []
    for e in wp.edges().vals():
        p0, p1, pm = e.positionAt(0.0), e.positionAt(1.0), e.positionAt(0.5)
        if max(abs(p0.y - y), abs(p1.y - y), abs(pm.y - y)) > 1e-4:
            continue
        rm = math.hypot(pm.x, pm.z)
        if rmin <= rm <= rmax:
            out.append(e)
    return out


# ---------------- main body of revolution ----------------
# back roll: circular arc tangent to the back plane at R_CREST passing through (R, CYL_LEN)
dy = T - CYL_LEN
rho = ((R - R_CREST) ** 2 + dy ** 2) / (2 * dy)
cy = T - rho
ang_mid = math.atan2(CYL_LEN - cy, R - R_CREST) * 0.5 + math.pi / 4
mid = (R_CREST + rho * math.cos(ang_mid), cy + rho * math.sin(ang_mid))
# inner dome: convex arc tangent to the back plane at R_CREST, down to the hub pocket rim
dr2 = R_CREST - DISH_R
dy2 = T - DISH_Y
rho2 = (dr2 ** 2 + dy2 ** 2) / (2 * dy2)
cy2 = T - rho2
a_end = math.atan2(DISH_Y - cy2, DISH_R - R_CREST)
a_mid2 = 0.5 * (math.pi / 2 + a_end)
mid2 = (R_CREST + rho2 * math.cos(a_mid2), cy2 + rho2 * math.sin(a_mid2))

prof = (
    cq.Workplane("XY")
    .moveTo(0, BOSS_FRONT)
    .lineTo(RB, BOSS_FRONT)
    .lineTo(RB, D_REC)
    .lineTo(RI, D_REC)
    .lineTo(RI, 0)
    .lineTo(R, 0)
    .lineTo(R, CYL_LEN)
    .threePointArc(mid, (R_CREST, T))
    .threePointArc(mid2, (DISH_R, DISH_Y))
    .lineTo(DISH_R, HUB_Y)
    .lineTo(0, HUB_Y)
    .close()
)
body = prof.revolve(360, (0, 0, 0), (0, 1, 0))

# edge treatment on the turned body
body = fillet_circ(body, R, CYL_LEN, ROLL_FIL)
body = fillet_circ(body, R, 0.0, RIM_OUT_FIL)
body = fillet_circ(body, RB, D_REC, BOSS_BASE_FIL)
body = fillet_circ(body, RB, BOSS_FRONT, BOSS_FRONT_FIL)
body = fillet_circ(body, DISH_R, DISH_Y, DISH_FIL)
body = fillet_circ(body, DISH_R, HUB_Y, HUB_FIL)

# ---------------- detent nubs (front edge of the rim wall) ----------------
for a in RIB_ANGS:
    ar = math.radians(a)
    cx, cz = (RI + 0.4) * math.cos(ar), (RI + 0.4) * math.sin(ar)
    nub = (
        cq.Workplane("XZ")
        .center(cx, cz)
        .circle(RIB_R)
        .extrude(-RIB_L)
    )
    body = body.union(nub)

# round the rim inner front edge together with the nubs
body = body.newObject(planar_edges(body, 0.0, RI - RIB_R - 0.5, RI + 0.5)).fillet(RIM_IN_FIL)

# ---------------- slot across the rim (one side only) ----------------
slot_len = R + 10.0 - SLOT_R0
slot = (
    cq.Workplane("XY")
    .box(SLOT_W, slot_len, SLOT_D + 5.0, centered=(True, False, False))
    .edges("|Y and >Z")
    .fillet(SLOT_FIL)
)
# local: X = across slot, Y = radial (outwards from SLOT_R0), Z = axial depth
slot = (
    slot.translate((0, SLOT_R0, -5.0))
    .rotate((0, 0, 0), (1, 0, 0), 90)   # local Y -> world Z, local Z -> world -Y
)
slot = slot.mirror("XZ")                 # axial depth now towards +Y
slot = slot.rotate((0, 0, 0), (0, 1, 0), -(SLOT_ANG - 90))
body = body.cut(slot)


# ---------------- latch tabs ----------------
def tab_solid(ang_deg):
    hb = TAB_BASE_W / 2.0
    rt = TAB_TIP_R
    c = TAB_P - rt                    # height of the tip-arc centre above the wall
    dist = math.hypot(hb, c)
    phi = math.atan2(-c, hb) + math.acos(rt / dist)   # tangent point angle
    tx, th = rt * math.cos(phi), c + rt * math.sin(phi)
    s = (
        cq.Workplane("XZ", origin=(0, TAB_FRONT, 0))
        .moveTo(-hb, RI + 1.5)
        .lineTo(-hb, RI)
        .lineTo(-tx, RI - th)
        .threePointArc((0, RI - TAB_P), (tx, RI - th))
        .lineTo(hb, RI)
        .lineTo(hb, RI + 1.5)
        .close()
        .extrude(-(D_REC - TAB_FRONT + 0.5))
    )
    return s.rotate((0, 0, 0), (0, 1, 0), -(ang_deg - 90))


for k in range(N_TABS):
    body = body.union(tab_solid(k * 360.0 / N_TABS))

# fillet the whole floor -> (rim wall + tabs) junction in one go
body = body.newObject(planar_edges(body, D_REC, RB + 2.0, R)).fillet(FLOOR_FIL)

# ---------------- through holes in the boss ----------------
pts = [(sx * HOLE_OFF, sz * HOLE_OFF) for sx in (-1, 1) for sz in (-1, 1)]
holes = cq.Workplane("XZ").pushPoints(pts).circle(HOLE_R).extrude(-(T + 2)).translate((0, -1, 0))
body = body.cut(holes)
hole_edges = [e for e in body.edges().vals()
              if e.geomType() == "CIRCLE" and abs(e.radius() - HOLE_R) < 0.05
              and abs(e.Center().y - BOSS_FRONT) < 0.05]
body = body.newObject(hole_edges).fillet(HOLE_FIL)

result = body
